import math
import cadquery as cq

# ------------------------------------------------------------------
# Toothed claw with a double-groove pulley head.
# Coordinates: pulley axis along +Y, front face of head at Y=0,
# pulley axis passes through X=0, Z=0.  Blade hangs down (-Z) and
# sweeps back (+Y); teeth are on the +X face of the blade.
# All driving dimensions are given in "reference units" U and scaled
# to millimetres by S.
# ------------------------------------------------------------------
S = 0.25  # mm per reference unit


def u(v):
    return v * S


# ---------------- head ----------------
R_HEAD = u(34.5)          # pulley / plate top radius
PLATE_T = u(8.3)          # front plate thickness (Y)
HEAD_BACK = u(30.3)       # back face of pulley (Y)
PLATE_BOT = u(-43.6)      # bottom of front plate (Z)
CHAMF_C = u(27.3)         # side chamfer plane offset (X - Y = C)
DISC_R = u(22.5)          # raised disc on front face
DISC_H = u(1.0)
CB_R = u(14.2)            # counterbore on front face
CB_D = u(1.2)              # counterbore depth below the raised disc face
HOLE_CHAMF = u(0.9)
HOLE_R = u(8.3)           # through bore

# pulley grooves (rounded U-grooves with a rounded ridge between them)
G1_Y0, G1_YB, G1_RB = u(8.5), u(12.8), u(27.6)   # groove 1: start Y, bottom Y, bottom radius
RIDGE_Y, RIDGE_DROP, RIDGE_HW = u(19.0), u(1.3), u(2.4)
G2_YB, G2_Y1, G2_RB = u(25.7), u(30.0), u(29.0)  # groove 2: bottom Y, end Y, bottom radius
FILL_DEPTH = u(1.6)        # remaining depth of the front groove where it is filled
FILL_START, FILL_SPAN = 100.0, 90.0   # filled sector (deg from +X towards -Z, about +Y)
BACK_DISC_R = u(21.0)
BACK_DISC_H = u(1.1)

# lower housing under the pulley
HOUS_Y1 = u(29.3)
HOUS_ZTOP = u(-19.0)
HOUS_X = (u(-27.0), u(24.0))                 # housing X range (under the pulley)
TAB_X, TAB_Y, TAB_Z = (u(18.0), u(29.0)), (u(8.0), u(16.3)), (u(-44.0), u(-22.0))
LATCH_X, LATCH_Y, LATCH_Z = (u(18.0), u(28.5)), (u(19.8), u(29.3)), (u(-39.0), u(-25.5))
LATCH_HOLE = (u(24.8), u(-31.1), u(2.5))   # Y, Z, radius (hole along X)

# ---------------- blade ----------------
BLADE_X_LEFT = u(-17.5)
TIP_X_LEFT = u(-10.5)
TOOTH_PITCH = u(6.9)
TOOTH_CREST = u(1.0)
FRONT_COL_Y = u(36.0)        # teeth in front of this Y start one pitch lower
TOOTH_TOP_Z = u(-79.5)
TOOTH_STEP_Z = u(-144.0)
UPPER_PEAK_X, UPPER_VALLEY_X = u(-5.5), u(-8.9)
BLADE_EDGE_R = u(2.0)
NECK_Y = (u(7.3), u(17.8))   # Y extent of the neck stem
NECK_EDGE_R = u(2.0)
LOWER_PEAK_X, LOWER_VALLEY_X = u(-2.5), u(-5.6)

# slot (teardrop, through X)
SLOT_TOP = (u(37.0), u(-88.5), u(10.0))   # Y, Z, r
SLOT_BOT = (u(39.8), u(-130.8), u(3.0))


def P(y, z):
    return (u(y), u(z))


# =================== front plate ===================
def plate_outline():
    return (
    cq.Workplane("XZ")
    .moveTo(R_HEAD, 0)
    .threePointArc((0, R_HEAD), (-R_HEAD, 0))
    .spline([P(-31.9, -17.5), P(-28.5, -29.0), P(-16.9, -43.6)],
            tangents=[(0, -1), (1, 0)], includeCurrent=True)
    .lineTo(u(16.9), PLATE_BOT)
    .spline([P(28.5, -29.0), P(31.9, -17.5), (R_HEAD, 0)],
            tangents=[(1, 0), (0, 1)], includeCurrent=True)
    .close()
    )


plate = plate_outline().extrude(-PLATE_T)

# 45 degree side chamfers (planar cuts X - Y > C and -X - Y > C)
big = u(400)
for sgn in (1, -1):
    tri = (
        cq.Workplane("XY")
        .workplane(offset=-big)
        .polyline([(sgn * (CHAMF_C - u(3)), -u(3)),
                   (sgn * (CHAMF_C + big), -u(3)),
                   (sgn * (CHAMF_C + big), big)])
        .close()
        .extrude(2 * big)
    )
    plate = plate.cut(tri)

# raised disc on the front face
disc = (cq.Workplane("XZ").circle(DISC_R).extrude(DISC_H))
plate = plate.union(disc)

# =================== pulley ===================
prof = (
    cq.Workplane("XY")
    .moveTo(0, PLATE_T - u(0.5))
    .lineTo(R_HEAD, PLATE_T - u(0.5))
    .lineTo(R_HEAD, G1_Y0)
    .threePointArc((G1_RB, G1_YB), (R_HEAD - RIDGE_DROP, RIDGE_Y - RIDGE_HW))
    .threePointArc((R_HEAD, RIDGE_Y), (R_HEAD - RIDGE_DROP, RIDGE_Y + RIDGE_HW))
    .threePointArc((G2_RB, G2_YB), (R_HEAD, G2_Y1))
    .lineTo(R_HEAD, HEAD_BACK)
    .lineTo(BACK_DISC_R, HEAD_BACK)
    .lineTo(BACK_DISC_R, HEAD_BACK + BACK_DISC_H)
    .lineTo(0, HEAD_BACK + BACK_DISC_H)
    .close()
)
pulley = prof.revolve(360, (0, 0, 0), (0, 1, 0))

# on the -X side the front groove is partly filled (shallow groove section)
groove_fill = (
    cq.Workplane("XY")
    .polyline([(G1_RB - u(0.3), G1_Y0), (R_HEAD - FILL_DEPTH, G1_Y0),
               (R_HEAD - FILL_DEPTH, RIDGE_Y - RIDGE_HW), (G1_RB - u(0.3), RIDGE_Y - RIDGE_HW)])
    .close()
    .revolve(FILL_SPAN, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 1, 0), FILL_START)
)
pulley = pulley.union(groove_fill)

# =================== lower housing, tab and latch ===================
def outline_prism(y0, y1):
    return plate_outline().extrude(-(y1 - y0)).translate((0, y0, 0))


def xyz_box(xr, yr, zr):
    return (cq.Workplane("XY")
            .box(xr[1] - xr[0], yr[1] - yr[0], zr[1] - zr[0], centered=False)
            .translate((xr[0], yr[0], zr[0])))


housing = (
    outline_prism(PLATE_T - u(0.5), HOUS_Y1)
    .intersect(xyz_box(HOUS_X, (-big, big), (-big, HOUS_ZTOP)))
    .edges("|Y").fillet(u(1.5))
)
tab = (xyz_box(TAB_X, TAB_Y, TAB_Z).edges("|Y").fillet(u(2.0))
       .intersect(outline_prism(PLATE_T - u(0.5), HOUS_Y1)))
latch = (xyz_box(LATCH_X, LATCH_Y, LATCH_Z).edges("|Y").fillet(u(3.0))
         .intersect(outline_prism(PLATE_T - u(0.5), HOUS_Y1 + u(1))))
housing = housing.union(tab).union(latch)
latch_hole = (
    cq.Workplane("YZ").workplane(offset=-big / 2)
    .center(LATCH_HOLE[0], LATCH_HOLE[1]).circle(LATCH_HOLE[2]).extrude(big)
)

head = plate.union(pulley).union(housing).cut(latch_hole)

# bore: counterbore + chamfer on front, through hole, chamfer on back
bore = cq.Workplane("XZ").workplane(offset=-big / 2).circle(HOLE_R).extrude(big)
cb_front = (cq.Workplane("XZ").workplane(offset=DISC_H + u(0.1)).circle(CB_R)
            .extrude(-(u(0.1) + CB_D)))
cb_floor_y = -DISC_H + CB_D
hole_csk = cq.Workplane("XY").add(cq.Solid.makeCone(
    HOLE_R + HOLE_CHAMF + u(0.1), HOLE_R - u(0.05), HOLE_CHAMF + u(0.15),
    cq.Vector(0, cb_floor_y - u(0.1), 0), cq.Vector(0, 1, 0)))
cb_front = cb_front.union(hole_csk)
back_face_y = HEAD_BACK + BACK_DISC_H
cb_back = cq.Workplane("XY").add(cq.Solid.makeCone(
    HOLE_R + HOLE_CHAMF + u(0.1), HOLE_R - u(0.05), HOLE_CHAMF + u(0.15),
    cq.Vector(0, back_face_y + u(0.1), 0), cq.Vector(0, -1, 0)))
head = head.cut(bore).cut(cb_front).cut(cb_back)

# =================== blade ===================
# side (YZ) outline of the neck + claw blade (front edge down to the tip,
# then the back edge up to the neck)
side_pts = [P(7.3, -69.1), P(9.4, -77.6), P(12.6, -86.1), P(16.5, -101.3),
             P(22.2, -122.0), P(24.5, -136.0), P(23.4, -157.5), P(20.3, -180.6),
             P(17.6, -195.0), P(19.0, -201.0), P(22.0, -203.0), P(25.5, -201.5),
             P(30.3, -195.9), P(39.6, -180.6), P(47.3, -165.2), P(52.6, -150.0),
             P(55.5, -135.0), P(56.6, -112.9), P(57.2, -92.0), P(56.0, -82.0),
             P(51.7, -74.4), P(46.4, -69.7), P(39.0, -66.5), P(30.5, -64.9),
             P(23.1, -62.3), P(18.9, -57.5), P(17.8, -51.1)]


def side_profile(x0, length):
    """Side (YZ) outline of neck + curved blade, extruded along +X."""
    return (
        cq.Workplane("YZ").workplane(offset=x0)
        .moveTo(*P(17.8, -38.0))
        .lineTo(*P(7.3, -38.0))
        .lineTo(*P(7.3, -55.0))
        .spline(side_pts, includeCurrent=True)
        .close()
        .extrude(length)
    )


def xz_prism(points):
    return cq.Workplane("XZ").workplane(offset=-big / 2).polyline(points).close().extrude(big)


side_raw = side_profile(-big / 2, big)

# concave transition arc below the neck block (centre NECK_ARC_C, radius NECK_ARC_R)
NECK_ARC_C, NECK_ARC_R = P(18.9, -71.9), u(24.4)
NECK_BLOCK_X = u(5.5)      # +X extent of the neck block under the head
NECK_X_IN = BLADE_X_LEFT + BLADE_EDGE_R + u(0.5)   # inner (-X) bound of the neck block
NECK_ARC_A0 = math.acos((NECK_BLOCK_X - NECK_ARC_C[0]) / NECK_ARC_R)
pts_arc_start = (NECK_ARC_C[0] + NECK_ARC_R * math.cos(NECK_ARC_A0),
                 NECK_ARC_C[1] + NECK_ARC_R * math.sin(NECK_ARC_A0))
pts_arc_mid = (NECK_ARC_C[0] + NECK_ARC_R * math.cos((NECK_ARC_A0 + math.pi) / 2),
               NECK_ARC_C[1] + NECK_ARC_R * math.sin((NECK_ARC_A0 + math.pi) / 2))
pts_arc_end = (NECK_ARC_C[0] - NECK_ARC_R, NECK_ARC_C[1])

# main slab of the blade: side outline limited in X by the -X face
# (straight, then tapering towards the tip) and the +X tooth-crest plane
slab_xz = (
    cq.Workplane("XZ").workplane(offset=-big / 2)
    .moveTo(UPPER_PEAK_X, u(-30))
    .lineTo(UPPER_PEAK_X, u(-212))
    .lineTo(TIP_X_LEFT, u(-212))
    .lineTo(TIP_X_LEFT, u(-207))
    .spline([P(-14.5, -175), P(-16.6, -145), (BLADE_X_LEFT, u(-115)), (BLADE_X_LEFT, u(-30))],
            tangents=[(-0.25, 1), (0, 1)], includeCurrent=True)
    .close()
    .extrude(big)
)
slab_base = side_raw.intersect(slab_xz)
minus_x_face = min(slab_base.faces().vals(), key=lambda f: f.Center().x)
slab_sharp = slab_base.newObject(minus_x_face.Edges()).fillet(BLADE_EDGE_R)
slab_round = slab_sharp.faces(">X").edges().fillet(BLADE_EDGE_R)


def z_box(z0, z1):
    return cq.Workplane("XY").box(big, big, z1 - z0, centered=(True, True, False)).translate((0, 0, z0))


# rounded knuckle above the teeth, square-edged toothed part below
# smooth (untoothed) zone: above TOOTH_TOP_Z, and one pitch lower on the
# front column (in front of the slot)
smooth_zone = z_box(TOOTH_TOP_Z, u(-30)).union(
    cq.Workplane("XY").box(big, big, TOOTH_PITCH, centered=(True, False, False))
    .translate((0, FRONT_COL_Y - big, TOOTH_TOP_Z - TOOTH_PITCH)))
slab = (slab_round.intersect(smooth_zone)
        .union(slab_sharp.cut(smooth_zone)))

# neck block below the head with a concave transition onto the blade face
neck = (
    cq.Workplane("XZ").workplane(offset=-NECK_Y[0])
    .polyline([(NECK_X_IN, u(-38.0)), (NECK_BLOCK_X, u(-38.0)), pts_arc_start])
    .threePointArc(pts_arc_mid, pts_arc_end)
    .lineTo(NECK_X_IN, pts_arc_end[1])
    .close()
    .extrude(-(NECK_Y[1] - NECK_Y[0]))
)


def _neck_edge(e):
    b = e.BoundingBox()
    return (abs(b.ymax - b.ymin) < 1e-6 and b.zmin < u(-38.5) and b.zmax > pts_arc_end[1] + u(0.5)
            and b.xmax > UPPER_PEAK_X - u(1.0))


neck = neck.newObject([e for e in neck.edges().vals() if _neck_edge(e)]).fillet(NECK_EDGE_R)

# lower blade section stands further out in +X
lower = side_raw.intersect(xz_prism([(UPPER_PEAK_X - u(1.5), TOOTH_STEP_Z),
                                     (LOWER_PEAK_X, TOOTH_STEP_Z),
                                     (LOWER_PEAK_X, u(-215)),
                                     (UPPER_PEAK_X - u(1.5), u(-215))]))

blade = slab.union(neck).union(lower)

# saw teeth: V-grooves cut into the +X face
z = TOOTH_TOP_Z
tooth_pts = [(u(30), TOOTH_TOP_Z), (UPPER_PEAK_X, TOOTH_TOP_Z)]
while z - TOOTH_PITCH > u(-212):
    if z - TOOTH_PITCH / 2 > TOOTH_STEP_Z:
        pk, vl = UPPER_PEAK_X, UPPER_VALLEY_X
    else:
        pk, vl = LOWER_PEAK_X, LOWER_VALLEY_X
    tooth_pts.append((pk, z - TOOTH_CREST))
    tooth_pts.append((vl, z - TOOTH_CREST - (TOOTH_PITCH - TOOTH_CREST) / 2))
    tooth_pts.append((pk, z - TOOTH_PITCH))
    z -= TOOTH_PITCH
tooth_pts.append((tooth_pts[-1][0], u(-215)))
tooth_pts.append((u(30), u(-215)))
blade = blade.cut(xz_prism(tooth_pts).cut(smooth_zone))

# teardrop slot through the blade
ty, tz, tr = SLOT_TOP
by, bz, br = SLOT_BOT
d = math.hypot(by - ty, bz - tz)
ang = math.atan2(bz - tz, by - ty)
phi = math.acos((tr - br) / d)
def pt(cy, cz, r, a):
    return (cy + r * math.cos(a), cz + r * math.sin(a))
a1 = ang + phi
a2 = ang - phi
p1t = pt(ty, tz, tr, a1)
p1b = pt(by, bz, br, a1)
p2t = pt(ty, tz, tr, a2)
p2b = pt(by, bz, br, a2)
slot = (
    cq.Workplane("YZ").workplane(offset=-big / 2)
    .moveTo(*p1t)
    .lineTo(*p1b)
    .threePointArc(pt(by, bz, br, ang), p2b)
    .lineTo(*p2t)
    .threePointArc(pt(ty, tz, tr, ang + math.pi), p1t)
    .close()
    .extrude(big)
)
blade = blade.cut(slot)

result = head.union(blade)

VIEW = {"azimuth": 45, "elevation": 26}
